"""Pipe-clamp half (saddle block): rounded rectangular block with a
cylindrical pipe seat across its width, a counterbored bolt hole at each end
(counterbore from the underside) and two blind mounting holes in the base."""
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 100.0          # overall length (Y)
W = 25.0           # overall width / thickness (X)
H = 38.45          # overall height (Z)
CORNER_R = 6.4     # fillet radius of the four vertical corner edges

BORE_R = 34.5      # pipe seat radius
BORE_Z_OFF = 3.25  # seat axis lies this far above the top face (clamping gap)

HOLE_D = 7.2       # bolt hole diameter (through, visible on top)
HOLE_E = 8.0       # bolt hole centre distance from each end
CB_D = 13.6        # counterbore diameter (from the underside)
CB_DEPTH = 15.0    # counterbore depth

BLIND_D = 7.4      # blind mounting holes in the underside
BLIND_E = 24.6     # their centre distance from each end
BLIND_DEPTH = 12.0

# ---------------- body ----------------
body = (
    cq.Workplane("XY")
    .box(W, L, H, centered=(True, True, False))
    .edges("|Z")
    .fillet(CORNER_R)
)

# pipe seat: cylinder whose axis runs along X, slightly above the top face
seat = (
    cq.Workplane("YZ")
    .workplane(offset=-W)
    .center(0, H + BORE_Z_OFF)
    .circle(BORE_R)
    .extrude(2 * W)
)
body = body.cut(seat)

# counterbored bolt holes, drilled from the underside right through
bolt_pts = [(0, -L / 2 + HOLE_E), (0, L / 2 - HOLE_E)]
body = (
    body.faces("<Z").workplane(centerOption="CenterOfBoundBox")
    .pushPoints(bolt_pts)
    .cboreHole(HOLE_D, CB_D, CB_DEPTH)
)

# blind mounting holes in the underside (under the seat)
blind_pts = [(0, -L / 2 + BLIND_E), (0, L / 2 - BLIND_E)]
body = (
    body.faces("<Z").workplane(centerOption="CenterOfBoundBox")
    .pushPoints(blind_pts)
    .hole(BLIND_D, BLIND_DEPTH)
)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
